import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 74.5          # width  (X)
H = 100.0         # height (Z)
D_LEFT = 21.6     # depth at -X side, measured from back plane (lip top) to front face
D_RIGHT = 4.6     # depth at +X side
LIP_H = 1.9       # height of the back lip
LIP_IN = 1.4      # lip inset from outer wall surface
T_WALL = 2.5      # side wall thickness
T_FRONT = 2.8     # front plate thickness
LEDGE_W = 0.6     # inner rebate (cover seat) width
LEDGE_D = 1.9     # inner rebate depth below lip top
R_CORNER = 2.2    # rounding of the box corners (front-view corners)
R_FRONT = 2.3     # fillet around the front face

HOLE_D = 6.0      # front recessed holes
HOLE_DEPTH = 2.7
HOLE_IN_X = 8.7   # hole inset from side edges (projected X)
HOLE_IN_Z = 9.0   # hole inset from top/bottom

PAD = 12.5        # corner pad size (from outer edge)
PAD_R = 3.0       # pad inner corner radius
PAD_HOLE_D = 3.2
PAD_HOLE_DEPTH = 10.0

BOSS_D = 5.5
BOSS_HOLE_D = 2.2
BOSS_LEN = 11.4   # from outer front face to boss tip (along face normal)
# boss axis positions where they meet the outer front face: (x, z), part centred at z=0
BOSS_POS = [(15.0, 10.0), (15.0, 28.3), (-12.6, 9.4), (-12.6, 27.7)]

BLK_X = (14.6, 30.2)
BLK_Z = (-31.8, -11.8)
BLK_OUT = 10.9    # block protrusion beyond back plane
BLK_HOLE_D = 2.0

SLOT_Y = (-11.4, -2.6)
SLOT_Z = (20.0, 30.4)

# ---------------- derived ----------------
ang = math.atan2(D_LEFT - D_RIGHT, W)
ca, sa = math.cos(ang), math.sin(ang)
n_in = cq.Vector(-sa, ca, 0)          # inward normal of front plate


def y_front(x):
    """outer front face y at given x"""
    return -D_LEFT + (D_LEFT - D_RIGHT) * (x + W / 2) / W


def y_front_in(x):
    return y_front(x) + T_FRONT / ca


# ---------------- outer body ----------------
body = (
    cq.Workplane("XY")
    .polyline([(-W / 2, -LIP_H), (W / 2, -LIP_H),
               (W / 2, y_front(W / 2)), (-W / 2, y_front(-W / 2))])
    .close()
    .extrude(H)
    .translate((0, 0, -H / 2))
)
# round the four corners seen in the front view (edges running along Y)
body = body.edges("|Y").fillet(R_CORNER)

# fillet the front face perimeter
front_edges = [e for e in body.edges().vals()
               if e.Center().y < -LIP_H - 0.5 and
               abs(e.Center().y - y_front(e.Center().x)) < 0.5]
body = body.newObject(front_edges).fillet(R_FRONT)

# lip at the back
lip = (
    cq.Workplane("XZ", origin=(0, 0, 0))
    .rect(W - 2 * LIP_IN, H - 2 * LIP_IN)
    .extrude(LIP_H)          # XZ normal is -Y -> extrude toward -Y
    .edges("|Y").fillet(max(R_CORNER - LIP_IN, 0.5))
)
body = body.union(lip)

# ---------------- cavity ----------------
xi0, xi1 = -W / 2 + T_WALL, W / 2 - T_WALL
cav = (
    cq.Workplane("XY")
    .polyline([(xi0, 1.0), (xi1, 1.0), (xi1, y_front_in(xi1)), (xi0, y_front_in(xi0))])
    .close()
    .extrude(H - 2 * T_WALL)
    .translate((0, 0, -H / 2 + T_WALL))
)
body = body.cut(cav)

# inner rebate around the opening (seat for a cover plate)
reb = cq.Workplane("XY").box(W - 2 * (T_WALL - LEDGE_W), LEDGE_D + 1.0, H - 2 * (T_WALL - LEDGE_W)) \
    .translate((0, (1.0 - LEDGE_D) / 2, 0))
body = body.cut(reb)

# ---------------- corner pads ----------------
for sx in (-1, 1):
    for sz in (-1, 1):
        x_out = sx * W / 2
        z_out = sz * H / 2
        x_in = sx * (W / 2 - PAD)
        z_in = sz * (H / 2 - PAD)
        xa, xb = sorted((x_out, x_in))
        za, zb = sorted((z_out, z_in))
        ylow = min(y_front_in(xa), y_front_in(xb)) - 0.5
        pad = (
            cq.Workplane("XY")
            .box(xb - xa, 0 - ylow, zb - za, centered=False)
            .translate((xa, ylow, za))
        )
        # round the inner corner edge (parallel to Y)
        pad = pad.edges("|Y").edges(
            cq.selectors.NearestToPointSelector((x_in, -5, z_in))).fillet(PAD_R)
        # keep only inside outer envelope: intersect with cavity region
        pad = pad.intersect(cav.union(reb))
        body = body.union(pad)
        # pad hole from the back
        hx = sx * (W / 2 - HOLE_IN_X)
        hz = sz * (H / 2 - HOLE_IN_Z)
        # stop short of the recess drilled from the front
        depth = min(PAD_HOLE_DEPTH, -(y_front(hx) + HOLE_DEPTH / ca) - 0.8)
        hole = cq.Solid.makeCylinder(PAD_HOLE_D / 2, depth + 1,
                                     cq.Vector(hx, 1.0, hz), cq.Vector(0, -1, 0))
        body = body.cut(cq.Workplane().add(hole))

# ---------------- bosses (perpendicular to front plate) ----------------
for (bx, bz) in BOSS_POS:
    p0 = cq.Vector(bx, y_front(bx), bz)          # axis meets the outer front face here
    start = p0 + n_in * (T_FRONT * 0.5)          # start inside the plate for a clean union
    boss = cq.Solid.makeCylinder(BOSS_D / 2, BOSS_LEN - T_FRONT * 0.5, start, n_in)
    body = body.union(cq.Workplane().add(boss))
    hole = cq.Solid.makeCylinder(BOSS_HOLE_D / 2, BOSS_LEN - T_FRONT + 0.5,
                                 p0 + n_in * (T_FRONT + 0.5), n_in)   # blind screw hole
    body = body.cut(cq.Workplane().add(hole))

# ---------------- block on the back ----------------
blk = (
    cq.Workplane("XY")
    .polyline([(BLK_X[0], y_front_in(BLK_X[0]) - 0.3), (BLK_X[1], y_front_in(BLK_X[1]) - 0.3),
               (BLK_X[1], BLK_OUT), (BLK_X[0], BLK_OUT)])
    .close()
    .extrude(BLK_Z[1] - BLK_Z[0])
    .translate((0, 0, BLK_Z[0]))
)
body = body.union(blk)
for (hx, hz) in ((BLK_X[0] + 2.2, BLK_Z[1] - 2.2), (BLK_X[1] - 2.2, BLK_Z[0] + 2.2)):
    h = cq.Solid.makeCylinder(BLK_HOLE_D / 2, 4.0, cq.Vector(hx, BLK_OUT + 0.5, hz), cq.Vector(0, -1, 0))
    body = body.cut(cq.Workplane().add(h))

# ---------------- slot in -X wall ----------------
slot = (
    cq.Workplane("XY")
    .box(T_WALL * 3, SLOT_Y[1] - SLOT_Y[0], SLOT_Z[1] - SLOT_Z[0], centered=False)
    .translate((-W / 2 - T_WALL, SLOT_Y[0], SLOT_Z[0]))
)
body = body.cut(slot)

# ---------------- front recessed holes ----------------
for sx in (-1, 1):
    for sz in (-1, 1):
        hx = sx * (W / 2 - HOLE_IN_X)
        hz = sz * (H / 2 - HOLE_IN_Z)
        p0 = cq.Vector(hx, y_front(hx), hz)
        rec = cq.Solid.makeCylinder(HOLE_D / 2, HOLE_DEPTH + 1.0, p0 - n_in * 1.0, n_in)
        body = body.cut(cq.Workplane().add(rec))

result = body
